import math
import cadquery as cq

# Hex head bolt standing on its head next to a matching hex nut.
# Both hexes have their corners on +/-X, both sit on z = 0.

# ---------------------------------------------------------------- parameters (mm)
# hex head bolt
head_af = 10.0            # head width across flats
head_h = 5.0              # head height
head_cham_d = 9.9         # diameter of the flat circle left by the head chamfer
cham_ang = 44.0           # chamfer angle of the hex corners (deg from the flat face)

d_major = 6.6             # thread major diameter
d_minor = 5.35            # thread minor (root) diameter
pitch = 1.65              # thread pitch (right hand, single start)
thread_len = 12.4         # length of the threaded shank above the head
thread_phase = 0.5        # crest height at +X above the head face, in pitches
tip_d = 4.9               # flat diameter at the chamfered tip
tip_ang = 45.0            # tip chamfer angle
root_flat = 0.02          # tiny land at the thread roots (keeps booleans transversal)

# hex nut
nut_af = 9.6              # nut width across flats
nut_h = 5.25              # nut height
nut_cham_d = 9.5          # flat circle diameter of the nut chamfer
nut_bore = 5.45           # internal thread minor diameter
nut_major = 6.6           # internal thread major diameter
nut_phase = 0.65          # internal thread phase, in pitches
nut_csk_d = 7.0           # countersink diameter at both nut faces
csk_ang = 45.0            # countersink half angle

# placement of the nut relative to the bolt axis
nut_dx = 15.8
nut_dy = -1.5


# ---------------------------------------------------------------- helpers
def revolve_z(pts):
    """Revolve a closed (r, z) profile about the Z axis; seam placed at -X."""
    return (
        cq.Workplane("XZ")
        .polyline(pts)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), 180)
    )


def chamfered_hex(af, h, cham_d, ang):
    """Hex prism (corners on +/-X) with conical chamfers top and bottom."""
    ac = af / math.cos(math.radians(30))
    prism = cq.Workplane("XY").polygon(6, ac).extrude(h)
    R = ac / 2 + 0.5
    rc = cham_d / 2
    dz = (R - rc) * math.tan(math.radians(ang))
    env = revolve_z([(0, 0), (rc, 0), (R, dz), (R, h - dz), (rc, h), (0, h)])
    return prism.intersect(env)


def helical_v(r_root, r_tip, p, z0, length, fill=0.995, sink=0.1):
    """V-thread ridge swept along a right-hand helix.

    The V flanks meet radius r_root at +/- fill*p/2 (almost touching the next
    turn); the profile is sunk `sink` beyond r_root so it overlaps the core
    (external thread) or opens into the bore (internal groove)."""
    hw = fill * p / 2
    hb = hw * 0.6
    r_base = r_root - sink if r_tip > r_root else r_root + sink
    helix = cq.Wire.makeHelix(p, length, r_root, center=cq.Vector(0, 0, z0))
    prof = (
        cq.Workplane("XZ")
        .polyline([
            (r_base, z0 - hb),
            (r_root, z0 - hw),
            (r_tip, z0),
            (r_root, z0 + hw),
            (r_base, z0 + hb),
        ])
        .close()
        .wires()
        .val()
    )
    return cq.Workplane("XY").add(cq.Solid.sweep(prof, [], helix, isFrenet=True))


def ring_profile(r_a, r_b, z0, z1, p):
    """Fallback thread (plain ring grooves): V profile points along z."""
    pts = []
    n = int(math.ceil((z1 - z0) / p)) + 1
    for k in range(n):
        pts.append((r_a, z0 + k * p))
        pts.append((r_b, z0 + (k + 0.5) * p))
    pts.append((r_a, z0 + n * p))
    return pts, z0 + n * p


def single_solid(wp):
    try:
        s = wp.val()
        return s.isValid() and len(s.Solids()) == 1
    except Exception:
        return False


def mean_sq(a, b):
    """Mean of r^2 over a linear ramp of r from a to b."""
    return (a * a + a * b + b * b) / 3.0


# ---------------------------------------------------------------- bolt
head = chamfered_hex(head_af, head_h, head_cham_d, cham_ang)

z_top = head_h + thread_len
r_min = d_minor / 2
r_maj = d_major / 2
r_big = r_maj + 0.5
tip_dz = (r_big - tip_d / 2) * math.tan(math.radians(tip_ang))
tip_env = revolve_z([
    (0, head_h - 0.5),
    (r_big, head_h - 0.5),
    (r_big, z_top - tip_dz),
    (tip_d / 2, z_top),
    (0, z_top),
])
core = (
    cq.Workplane("XY")
    .workplane(offset=head_h - 0.3)
    .circle(r_min + root_flat)
    .extrude(thread_len + 0.3)
    .intersect(tip_env)
)
blank_vol = head.union(core).val().Volume()
# volume the thread ridge should add (V ridge over the usable length)
ridge_vol = math.pi * (mean_sq(r_min, r_maj) - r_min ** 2) * (thread_len - 1.0)


def bolt_helical(phase):
    z_start = head_h + (phase - 1.0) * pitch          # ridge starts inside the head
    ridge = helical_v(r_min, r_maj, pitch, z_start, z_top - z_start + pitch)
    return head.union(core.union(ridge.intersect(tip_env)))


def bolt_rings():
    z_base = head_h - 0.3
    pts, z_end = ring_profile(r_min, r_maj, head_h, z_top, pitch)
    shank = revolve_z([(0, z_base), (r_min, z_base)] + pts + [(0, z_end)])
    return head.union(shank.intersect(tip_env))


bolt = None
for ph in (thread_phase, thread_phase - 0.05, thread_phase - 0.1, thread_phase + 0.05):
    try:
        cand = bolt_helical(ph)
    except Exception:
        continue
    if single_solid(cand):
        added = cand.val().Volume() - blank_vol
        if 0.6 * ridge_vol < added < 1.6 * ridge_vol:
            bolt = cand
            break
if bolt is None:
    bolt = bolt_rings()

# ---------------------------------------------------------------- nut
rb = nut_bore / 2
rM = nut_major / 2
rcs = nut_csk_d / 2
cdz = (rcs + 1.0) / math.tan(math.radians(csk_ang))

nut_blank = chamfered_hex(nut_af, nut_h, nut_cham_d, cham_ang)
nut_blank = nut_blank.cut(
    cq.Workplane("XY").workplane(offset=-1.0).circle(rb - root_flat).extrude(nut_h + 2.0)
)
csk_bot = revolve_z([(0, -1.0), (rcs + 1.0, -1.0), (0, -1.0 + cdz)])
csk_top = revolve_z([(0, nut_h + 1.0), (rcs + 1.0, nut_h + 1.0), (0, nut_h + 1.0 - cdz)])
nut_blank = nut_blank.cut(csk_bot).cut(csk_top)
nut_blank_vol = nut_blank.val().Volume()
# volume the internal groove should remove (between the two countersinks)
groove_vol = math.pi * (mean_sq(rb, rM) - rb ** 2) * (nut_h - 2 * (rcs - rb))


def nut_helical(phase):
    nz0 = (phase - 2.0) * pitch
    groove = helical_v(rb, rM, pitch, nz0, nut_h - nz0 + 2 * pitch)
    # trim the groove so its ends lie inside the countersink cones
    slab = cq.Workplane("XY").workplane(offset=0.1).rect(4 * rM, 4 * rM).extrude(nut_h - 0.2)
    return nut_blank.cut(groove.intersect(slab))


def nut_rings():
    ipts, iz_end = ring_profile(rb, rM, -1.0, nut_h + 1.0, pitch)
    return nut_blank.cut(revolve_z([(0, -1.0)] + ipts + [(0, iz_end)]))


nut = None
for ph in (nut_phase, nut_phase - 0.05, nut_phase - 0.1, nut_phase - 0.15, nut_phase - 0.2):
    try:
        cand = nut_helical(ph)
    except Exception:
        continue
    if single_solid(cand):
        removed = nut_blank_vol - cand.val().Volume()
        if 0.6 * groove_vol < removed < 1.6 * groove_vol:
            nut = cand
            break
if nut is None:
    nut = nut_rings()

nut = nut.translate((nut_dx, nut_dy, 0))

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound([bolt.val(), nut.val()])])

VIEW = {"azimuth": 45, "elevation": 26}
